import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R_DISK = 200.0          # outer radius of the plate
T_PLATE = 6.8           # plate thickness
EDGE_T = 2.2            # height of the vertical rim face
RIM_R0 = 193.6          # radius where the chamfered underside of the rim starts
SEAM_ANGLE = 135.0      # where the revolve seam sits (cosmetic only)

# shallow spot-face recess around the hub on top
HUB_R = 29.3
HUB_DEPTH = 0.4
BORE_R = 17.2           # central bore
BORE_BOSS_R = 18.2      # short tube under the bore
BORE_BOSS_H = 1.8

# 4 small holes around the bore
HUB_HOLE_PCD_R = 23.0
HUB_HOLE_D = 5.8
HUB_HOLE_BOSS_R = 4.0
HUB_HOLE_BOSS_H = 1.8

# 8 perimeter holes (pattern centre slightly off the disc axis, as measured)
PER_HOLE_R = 186.8
PER_HOLE_D = 6.5
PER_BOSS_R_TOP = 4.7     # tapered (conical) boss under each perimeter hole
PER_BOSS_R_BOT = 3.9
PER_BOSS_H = 1.1
PER_CX, PER_CY = 1.45, -0.5
N_PER = 8

# 8 arc ribs on top (pattern centre slightly off the disc axis, as measured)
RIB_R = 187.2           # centre-line radius of ribs
RIB_W = 2.2             # radial width
RIB_H = 3.6             # height above plate top
RIB_HALF_SPAN = 9.4     # deg, half angular length
RIB_START = 22.5        # deg, angle of first rib
RIB_CX, RIB_CY = -4.1, -0.6
N_RIB = 8

# ---------------- base plate (revolved profile) ----------------
rise = T_PLATE - EDGE_T
prof = (
    cq.Workplane("XZ")
    .moveTo(0, 0)
    .lineTo(RIM_R0, 0)
    .lineTo(R_DISK, rise)          # bottom rim chamfer
    .lineTo(R_DISK, T_PLATE)
    .lineTo(0, T_PLATE)
    .close()
)
plate = prof.revolve(360, (0, 0, 0), (0, 1, 0)).rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE)


# short bosses on the underside: bore tube, 4 hub-hole bosses, 8 perimeter-hole bosses
hub_pts = [
    (HUB_HOLE_PCD_R * math.cos(math.radians(a)), HUB_HOLE_PCD_R * math.sin(math.radians(a)))
    for a in (0, 90, 180, 270)
]
per_pts = [
    (PER_CX + PER_HOLE_R * math.cos(math.radians(360.0 / N_PER * i)),
     PER_CY + PER_HOLE_R * math.sin(math.radians(360.0 / N_PER * i)))
    for i in range(N_PER)
]
under = cq.Workplane("XY").workplane(offset=1.0).circle(BORE_BOSS_R).extrude(-1.0 - BORE_BOSS_H)
under = under.union(
    cq.Workplane("XY").workplane(offset=1.0)
    .pushPoints(hub_pts).circle(HUB_HOLE_BOSS_R).extrude(-1.0 - HUB_HOLE_BOSS_H)
)
for (px, py) in per_pts:
    cone = cq.Solid.makeCone(
        PER_BOSS_R_BOT, PER_BOSS_R_TOP + (PER_BOSS_R_TOP - PER_BOSS_R_BOT) * 0.5 / PER_BOSS_H,
        PER_BOSS_H + 0.5, cq.Vector(px, py, -PER_BOSS_H), cq.Vector(0, 0, 1),
    )
    under = under.union(cq.Workplane("XY").add(cone))
plate = plate.union(under)


# thin arc ribs standing on the top face
def rib(angle_deg):
    a0 = math.radians(angle_deg - RIB_HALF_SPAN)
    a1 = math.radians(angle_deg + RIB_HALF_SPAN)
    am = math.radians(angle_deg)
    ri = RIB_R - RIB_W / 2
    ro = RIB_R + RIB_W / 2

    def p(r, a):
        return (RIB_CX + r * math.cos(a), RIB_CY + r * math.sin(a))

    return (
        cq.Workplane("XY").workplane(offset=T_PLATE - 0.5)
        .moveTo(*p(ri, a0))
        .lineTo(*p(ro, a0))
        .threePointArc(p(ro, am), p(ro, a1))
        .lineTo(*p(ri, a1))
        .threePointArc(p(ri, am), p(ri, a0))
        .close()
        .extrude(RIB_H + 0.5)
    )


for i in range(N_RIB):
    plate = plate.union(rib(RIB_START + 360.0 / N_RIB * i))

# through holes
cut_h = 50.0
bore = cq.Workplane("XY").workplane(offset=-20).circle(BORE_R).extrude(cut_h)
hub_holes = cq.Workplane("XY").workplane(offset=-20).pushPoints(hub_pts).circle(HUB_HOLE_D / 2).extrude(cut_h)
per_holes = cq.Workplane("XY").workplane(offset=-20).pushPoints(per_pts).circle(PER_HOLE_D / 2).extrude(cut_h)
spot = cq.Workplane("XY").workplane(offset=T_PLATE - HUB_DEPTH).circle(HUB_R).extrude(5.0)
plate = plate.cut(spot).cut(bore).cut(hub_holes).cut(per_holes)

result = plate

VIEW = {"azimuth": 45, "elevation": 26}
